import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 70.0          # width  (X)
H = 100.0         # height (Z)
D = 30.0          # depth  (Y); front face at -Y is closed, back (+Y) is open
T = 3.5           # side / top / bottom wall thickness
T_FRONT = 8.4     # front panel thickness (floor of the cavity)
R_EDGE = 3.2      # round on the four edges running along Y
R_FRONT = 3.0     # round on the front face perimeter
R_IN = 3.0        # inner cavity corner round

# top slot (through the top wall)
SLOT_W = 15.8     # along X
SLOT_D = 6.6      # along Y
SLOT_Y = 6.1      # slot centre (Y)
SLOT_R = 0.8

# corner screw bosses
BOSS = 10.0       # boss extent from the inner walls
BOSS_R = 5.5      # rounded inner corner (concentric with the hole)
BOSS_TOP_Y = 10.8 # boss face position (below the rim at D/2)
HOLE_D = 4.2
HOLE_DEPTH = 10.0

# vertical post on the floor, under the top wall
POST_W = 5.3      # along X
POST_T = 4.6      # along Y (off the floor)
POST_Z0 = 0.0     # lower end of the post

# bottom ledge (block along the bottom wall, on the floor)
LEDGE_H = 10.0     # height above the bottom wall inner face
LEDGE_T = 5.7     # thickness off the floor

# cable notch in the bottom wall at the open back edge
NOTCH_W = 6.0
NOTCH_D = 5.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
xi = W / 2 - T                 # inner wall X
zi = H / 2 - T                 # inner wall Z
y_floor = -D / 2 + T_FRONT     # cavity floor
y_rim = D / 2

# ---------------- outer shell ----------------
outer = cq.Workplane("XY").box(W, D, H)
outer = outer.edges("|Y").fillet(R_EDGE)
outer = outer.faces("<Y").edges().fillet(R_FRONT)

cavity = (
    cq.Workplane("XZ", origin=(0, y_rim + 1, 0))
    .rect(2 * xi, 2 * zi)
    .extrude(y_rim + 1 - y_floor)
    .edges("|Y").fillet(R_IN)
)
body = outer.cut(cavity)

# ---------------- corner bosses ----------------
boss_len = BOSS_TOP_Y - y_floor
hx = xi - (BOSS - BOSS_R)     # hole centre X (positive corner)
hz = zi - (BOSS - BOSS_R)     # hole centre Z
for sx in (-1, 1):
    for sz in (-1, 1):
        cx = sx * (xi - BOSS / 2)
        cz = sz * (zi - BOSS / 2)
        b = (
            cq.Workplane("XZ", origin=(0, BOSS_TOP_Y, 0))
            .center(cx, cz)
            .rect(BOSS, BOSS)
            .extrude(boss_len)
        )
        b = b.edges("|Y").edges(
            cq.selectors.NearestToPointSelector((cx - sx * BOSS, 0, cz - sz * BOSS))
        ).fillet(BOSS_R - 0.01)
        body = body.union(b)

body = body.cut(
    cq.Workplane("XZ", origin=(0, BOSS_TOP_Y, 0))
    .pushPoints([(sx * hx, sz * hz) for sx in (-1, 1) for sz in (-1, 1)])
    .circle(HOLE_D / 2)
    .extrude(HOLE_DEPTH)
)

# ---------------- bottom ledge ----------------
ledge = cq.Workplane("XY").box(2 * xi, LEDGE_T, LEDGE_H).translate(
    (0, y_floor + LEDGE_T / 2, -zi + LEDGE_H / 2)
)
body = body.union(ledge)

# ---------------- vertical post ----------------
post_len = zi - POST_Z0
post = cq.Workplane("XY").box(POST_W, POST_T, post_len).translate(
    (0, y_floor + POST_T / 2, POST_Z0 + post_len / 2)
)
body = body.union(post)

# ---------------- top slot ----------------
slot = (
    cq.Workplane("XY", origin=(0, 0, H / 2 + 1))
    .center(0, SLOT_Y)
    .rect(SLOT_W, SLOT_D)
    .extrude(-(T + 2))
    .edges("|Z").fillet(SLOT_R)
)
body = body.cut(slot)

# ---------------- bottom notch ----------------
notch = cq.Workplane("XY").box(NOTCH_W, NOTCH_D * 2, T * 2).translate((0, y_rim, -H / 2))
body = body.cut(notch)

result = body
